import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 142.0          # base length (X)
W = 59.0           # base depth (Y)
T = 9.3            # base thickness
R_FL = 9.0         # base corner radius front-left
R_FR = 9.5         # base corner radius front-right
R_BR = 10.0        # base corner radius back-right

# watch / accessory tower (left)
TW_X = 56.2        # tower length in X
TW_Y0 = 22.6       # tower front face Y
TW_H = 46.7        # tower top height (from base bottom)
TW_R = 13.2        # tower corner radius (also base back-left corner)
IN_X0, IN_X1 = 5.3, 51.0     # inner stadium pocket X range
IN_Y0, IN_Y1 = 31.5, 53.6    # inner stadium pocket Y range
REC_D = 28.8       # circular recess dia on tower front
REC_Z = 24.2       # recess centre height
REC_DEPTH = 6.0
PIN_D = 3.0        # small through hole above recess centre
PIN_Z = 36.1

# slot in front of tower
SL_X0, SL_X1 = 7.0, 49.4
SL_Y0, SL_Y1 = 10.5, 20.2
SL_DEPTH = 3.0
SL_FILLET = 2.5

# phone plate
P_X0 = 62.3        # plate left edge
P_W = L - P_X0     # plate width (flush with base right end)
P_TILT = 22.5      # degrees back from vertical
P_T = 11.6         # plate thickness
P_Y0 = 19.8        # front face Y at base top
P_TOPZ = 101.4     # height of top-front edge
P_CR = 6.6         # plate top corner radius
HOLE_D = 72.0      # charger hole diameter at the front face
HOLE_D2 = 67.2     # hole diameter at the back face (tapered bore)
HOLE_TOP_GAP = -0.5  # hole just breaks through the top edge (front)
CH_W = 20.0        # cable channel width (back of plate)
CH_D = 6.5         # cable channel depth

# phone rest pocket + lip
PK_X0, PK_X1 = 64.6, 138.0
PK_Y0, PK_Y1 = 5.0, 21.6
PK_R = 5.5
PK_DEPTH = 1.5
LIP_X0, LIP_X1 = 77.5, 126.8
LIP_H = 5.2
LIP_Y0, LIP_Y1 = 0.0, 3.0

# cable holes
SQ_Y0, SQ_Y1 = 37.2, 45.5     # square hole behind plate (X = channel width)
KH_X0, KH_X1 = 7.4, 35.0      # keyhole (watch cable) in the tower floor
KH_Y = 42.1                   # keyhole centre line
KH_W = 7.3                    # keyhole lobe width
KH_LOBE = 12.2                # length of each rounded lobe
KH_NECK = 4.8                 # neck width between the lobes
BP_Y0, BP_Y1, BP_DEPTH = 30.0, 51.0, 4.0   # pocket in base top behind plate (cable)

# underside
UR_X0, UR_X1 = 59.5, 139.5    # shallow recess under plate section
UR_Y0, UR_Y1 = 2.5, 56.5
UR_DEPTH = 0.6
UP_W = 30.0                   # pocket around square hole (X width, centred)
UP_Y0, UP_Y1 = 29.0, 50.0
UP_DEPTH = 2.5
GR_R = 2.5                    # cable groove to back edge (under plate centre)
TG_X0, TG_X1 = 30.0, 38.0     # watch cable channel under tower
TG_Y0 = 23.5
TR_X0, TR_X1 = 22.0, 38.0     # small pocket at the channel start
TR_Y1 = 30.5
TG_DEPTH = 2.0

a = math.radians(P_TILT)


def rrect(x0, y0, x1, y1, r_bl, r_br, r_tr, r_tl):
    """Rounded rectangle wire on XY plane with individual corner radii."""
    wp = cq.Workplane("XY").moveTo(x0 + r_bl, y0).lineTo(x1 - r_br, y0)
    if r_br > 0:
        wp = wp.radiusArc((x1, y0 + r_br), -r_br)
    wp = wp.lineTo(x1, y1 - r_tr)
    if r_tr > 0:
        wp = wp.radiusArc((x1 - r_tr, y1), -r_tr)
    wp = wp.lineTo(x0 + r_tl, y1)
    if r_tl > 0:
        wp = wp.radiusArc((x0, y1 - r_tl), -r_tl)
    wp = wp.lineTo(x0, y0 + r_bl)
    if r_bl > 0:
        wp = wp.radiusArc((x0 + r_bl, y0), -r_bl)
    return wp.close()


# ---------------- base ----------------
base = rrect(0, 0, L, W, R_FL, R_FR, R_BR, TW_R).extrude(T)

# ---------------- tower ----------------
# left end: rounded corners flush with the base; right end: full semicircle
tw_half = (W - TW_Y0) / 2
tower = (cq.Workplane("XY")
         .moveTo(TW_R, TW_Y0)
         .lineTo(TW_X - tw_half, TW_Y0)
         .threePointArc((TW_X, TW_Y0 + tw_half), (TW_X - tw_half, W))
         .lineTo(TW_R, W)
         .radiusArc((0, W - TW_R), -TW_R)
         .lineTo(0, TW_Y0 + TW_R)
         .radiusArc((TW_R, TW_Y0), -TW_R)
         .close()
         .extrude(TW_H))
body = base.union(tower)

# inner stadium pocket of the tower
in_len = IN_X1 - IN_X0
in_w = IN_Y1 - IN_Y0
pocket = (cq.Workplane("XY").workplane(offset=T)
          .center((IN_X0 + IN_X1) / 2, (IN_Y0 + IN_Y1) / 2)
          .slot2D(in_len, in_w).extrude(TW_H))
body = body.cut(pocket)

# circular recess on tower front + small through hole
rec = (cq.Workplane("XZ", origin=(0, TW_Y0, 0)).center(TW_X / 2, REC_Z)
       .circle(REC_D / 2).extrude(-REC_DEPTH))
body = body.cut(rec)
pin = (cq.Workplane("XZ", origin=(0, TW_Y0, 0)).center(TW_X / 2, PIN_Z)
       .circle(PIN_D / 2).extrude(-(IN_Y0 - TW_Y0 + 1)))
body = body.cut(pin)

# keyhole through the tower floor
kh_a = KH_X0 + KH_LOBE / 2
kh_b = KH_X1 - KH_LOBE / 2
kh = (cq.Workplane("XY").workplane(offset=-1)
      .pushPoints([(kh_a, KH_Y), (kh_b, KH_Y)])
      .slot2D(KH_LOBE, KH_W).extrude(T + 2))
kh = kh.union(cq.Workplane("XY").workplane(offset=-1)
              .center((kh_a + kh_b) / 2, KH_Y)
              .rect(kh_b - kh_a, KH_NECK).extrude(T + 2))
body = body.cut(kh)

# slot in front of tower
slot = (cq.Workplane("XY").workplane(offset=T - SL_DEPTH)
        .center((SL_X0 + SL_X1) / 2, (SL_Y0 + SL_Y1) / 2)
        .slot2D(SL_X1 - SL_X0, SL_Y1 - SL_Y0).extrude(SL_DEPTH + 1))
slot = slot.faces("<Z").edges().fillet(SL_FILLET)
body = body.cut(slot)

# phone rest pocket (cut before the plate is added)
pk = rrect(PK_X0, PK_Y0, PK_X1, PK_Y1, PK_R, PK_R, PK_R, PK_R).extrude(PK_DEPTH + 1)
pk = pk.translate((0, 0, T - PK_DEPTH))
body = body.cut(pk)

# ---------------- inclined plate ----------------
s_top = (P_TOPZ - T) / math.cos(a)        # slope length above base top
s_ext = T / math.cos(a) * 0.95            # extension down into the base
plate = (cq.Workplane("XY")
         .box(P_W, s_top + s_ext, P_T, centered=False)
         .translate((0, -s_ext, -P_T)))
plate = plate.edges("|Z").edges(">Y").fillet(P_CR)
s_c = s_top - HOLE_TOP_GAP - HOLE_D / 2
k_taper = (HOLE_D - HOLE_D2) / 2 / P_T
cone = cq.Solid.makeCone(HOLE_D / 2 + k_taper, HOLE_D2 / 2 - k_taper, P_T + 2,
                         cq.Vector(P_W / 2, s_c, 1), cq.Vector(0, 0, -1))
plate = plate.cut(cq.Workplane("XY").add(cone))
plate = (plate.rotate((0, 0, 0), (1, 0, 0), 90 - P_TILT)
         .translate((P_X0, P_Y0, T)))
# cable channel tool on the back of the plate (runs down into the base pocket)
ch_back = 12.0
channel = (cq.Workplane("XY")
           .box(CH_W, s_c + 12.0, CH_D + ch_back, centered=False)
           .translate((P_W / 2 - CH_W / 2, -12.0, -P_T - ch_back))
           .rotate((0, 0, 0), (1, 0, 0), 90 - P_TILT)
           .translate((P_X0, P_Y0, T)))
channel = channel.intersect(
    cq.Workplane("XY").box(L + 20, W + 40, 200, centered=(True, True, False))
    .translate((L / 2, W / 2, T - BP_DEPTH)))
# trim anything of the plate foot that would poke out below the base
keep = cq.Workplane("XY").box(L + 20, W + 40, 200, centered=(True, True, False)) \
    .translate((L / 2, W / 2, 0))
plate = plate.intersect(keep)
body = body.union(plate)

# front lip (low arch)
lip = (cq.Workplane("XZ", origin=(0, LIP_Y0, 0))
       .moveTo(LIP_X0, T - 0.5).lineTo(LIP_X0, T)
       .threePointArc(((LIP_X0 + LIP_X1) / 2, T + LIP_H), (LIP_X1, T))
       .lineTo(LIP_X1, T - 0.5).close()
       .extrude(-(LIP_Y1 - LIP_Y0)))
lip = lip.faces(">Z").edges("not |Y").fillet((LIP_Y1 - LIP_Y0) / 2 - 0.05)
body = body.union(lip)

# square cable hole through the base behind the plate
sq = (cq.Workplane("XY").workplane(offset=-1)
      .center(P_X0 + P_W / 2, (SQ_Y0 + SQ_Y1) / 2)
      .rect(CH_W, SQ_Y1 - SQ_Y0).extrude(T + 2))
body = body.cut(sq)

# pocket in base top behind the plate (continuation of the cable channel)
bp = (cq.Workplane("XY").workplane(offset=T - BP_DEPTH)
      .center(P_X0 + P_W / 2, (BP_Y0 + BP_Y1) / 2)
      .rect(CH_W, BP_Y1 - BP_Y0).extrude(BP_DEPTH + 1))
body = body.cut(bp).cut(channel)

# ---------------- underside ----------------
ur = rrect(UR_X0, UR_Y0, UR_X1, UR_Y1, 1.0, R_FR - 2.5, R_BR - 2.5, 1.0) \
    .extrude(UR_DEPTH + 0.5).translate((0, 0, -0.5))
body = body.cut(ur)
up = (cq.Workplane("XY").workplane(offset=-0.5)
      .center(P_X0 + P_W / 2, (UP_Y0 + UP_Y1) / 2)
      .rect(UP_W, UP_Y1 - UP_Y0).extrude(UR_DEPTH + UP_DEPTH + 0.5))
body = body.cut(up)
gr = (cq.Workplane("XZ", origin=(0, (UP_Y0 + UP_Y1) / 2, 0))
      .center(P_X0 + P_W / 2, UR_DEPTH).circle(GR_R).extrude(-(W - (UP_Y0 + UP_Y1) / 2 + 1)))
body = body.cut(gr)
tg = (cq.Workplane("XY").workplane(offset=-0.5)
      .center((TG_X0 + TG_X1) / 2, (TG_Y0 + W + 1) / 2)
      .rect(TG_X1 - TG_X0, W + 1 - TG_Y0).extrude(TG_DEPTH + 0.5))
body = body.cut(tg)
tr = (cq.Workplane("XY").workplane(offset=-0.5)
      .center((TR_X0 + TR_X1) / 2, (TG_Y0 + TR_Y1) / 2)
      .rect(TR_X1 - TR_X0, TR_Y1 - TG_Y0).extrude(TG_DEPTH + 0.5))
body = body.cut(tr)

result = body
